import math
import cadquery as cq

# Formed (swaged) tube: two plain tube ends of equal diameter joined by a
# necked-down waist.  Short, steep, well rounded shoulder on the front (-Y)
# end, long gentle taper towards the rear (+Y) end.  Bore follows the outside,
# both ends open.  Axis along Y.

# ---------------- driving dimensions (mm) ----------------
R_OUT = 12.15          # outer radius of both plain tube ends
WALL = 2.0             # wall thickness of the plain tube ends
WALL_NECK = 1.87       # wall thickness at the neck (drawn down slightly thinner)
LENGTH = 125.6         # overall length along Y

NECK_Y = 52.5          # axial position of the narrowest point (from front end)
NECK_R = 6.95          # outer radius at the narrowest point

FRONT_SLOPE = 0.85     # dr/dy of the conical part of the front shoulder
FRONT_CONCAVE = 3.3    # concave radius blending the front shoulder into the neck
FRONT_CONVEX = 9.0     # convex radius blending the front tube into the shoulder

REAR_SLOPE = 0.35      # dr/dy of the conical part of the rear taper
REAR_CONCAVE = 13.5    # concave radius blending the neck into the rear taper
REAR_CONVEX = 17.0     # convex radius blending the rear taper into the rear tube

SEAM_ANGLE = 135.0     # cosmetic: where the revolve seam sits around the axis

VIEW = {"azimuth": 45, "elevation": 26}


def profile_segments(r_tube, r_neck, r_front_cvx, r_front_ccv, r_rear_ccv, r_rear_cvx):
    """Half-section generator in (r, y): plain tube of radius r_tube, convex
    round, conical front shoulder, two concave rounds meeting tangentially at
    the neck (r_neck at NECK_Y), conical rear taper, convex round, plain tube."""
    y0 = -LENGTH / 2.0
    y1 = y0 + LENGTH
    yn = y0 + NECK_Y

    th1 = math.atan(FRONT_SLOPE)
    th3 = math.atan(REAR_SLOPE)

    # ---- front side -------------------------------------------------
    n1 = (-math.cos(th1), -math.sin(th1))          # normal towards the axis
    d1 = (math.sin(th1), -math.cos(th1))           # runs towards -Y, r grows
    ca = (r_neck + r_front_ccv, yn)                # concave centre (outside)
    ta = (ca[0] + r_front_ccv * n1[0], ca[1] + r_front_ccv * n1[1])
    s = (r_tube - r_front_cvx + r_front_cvx * math.cos(th1) - ta[0]) / math.sin(th1)
    t1 = (ta[0] + s * d1[0], ta[1] + s * d1[1])
    c1 = (t1[0] + r_front_cvx * n1[0], t1[1] + r_front_cvx * n1[1])

    # ---- rear side --------------------------------------------------
    n3 = (-math.cos(th3), math.sin(th3))
    d3 = (math.sin(th3), math.cos(th3))            # runs towards +Y, r grows
    cb = (r_neck + r_rear_ccv, yn)
    tb = (cb[0] + r_rear_ccv * n3[0], cb[1] + r_rear_ccv * n3[1])
    s = (r_tube - r_rear_cvx + r_rear_cvx * math.cos(th3) - tb[0]) / math.sin(th3)
    t3 = (tb[0] + s * d3[0], tb[1] + s * d3[1])
    c3 = (t3[0] + r_rear_cvx * n3[0], t3[1] + r_rear_cvx * n3[1])

    def on_arc(c, rad, ang):
        return (c[0] + rad * math.cos(ang), c[1] + rad * math.sin(ang))

    return [
        ("L", (r_tube, y0), (r_tube, c1[1])),
        ("A", (r_tube, c1[1]), on_arc(c1, r_front_cvx, th1 / 2.0), t1),
        ("L", t1, ta),
        ("A", ta, on_arc(ca, r_front_ccv, math.pi + th1 / 2.0), (r_neck, yn)),
        ("A", (r_neck, yn), on_arc(cb, r_rear_ccv, math.pi - th3 / 2.0), tb),
        ("L", tb, t3),
        ("A", t3, on_arc(c3, r_rear_cvx, -th3 / 2.0), (r_tube, c3[1])),
        ("L", (r_tube, c3[1]), (r_tube, y1)),
    ]


outer = profile_segments(R_OUT, NECK_R, FRONT_CONVEX, FRONT_CONCAVE,
                         REAR_CONCAVE, REAR_CONVEX)
# bore: parallel to the outside (same slopes), full wall in the plain tubes,
# slightly thinned wall in the drawn-down neck
inner = profile_segments(R_OUT - WALL, NECK_R - WALL_NECK, FRONT_CONVEX - WALL,
                         FRONT_CONCAVE + WALL_NECK, REAR_CONCAVE + WALL_NECK,
                         REAR_CONVEX - WALL)

# closed half-section: outside forward, rear end face, bore backward, front end face
wp = cq.Workplane("XY").moveTo(*outer[0][1])
for sg in outer:
    if sg[0] == "L":
        wp = wp.lineTo(*sg[2])
    else:
        wp = wp.threePointArc(sg[2], sg[3])
wp = wp.lineTo(*inner[-1][2])
for sg in reversed(inner):
    if sg[0] == "L":
        wp = wp.lineTo(*sg[1])
    else:
        wp = wp.threePointArc(sg[2], sg[1])
wp = wp.close()

body = wp.revolve(360, (0, 0, 0), (0, 1, 0))
# turn the revolve seam to the lower rear side, away from the main viewing direction
result = body.rotate((0, 0, 0), (0, 1, 0), SEAM_ANGLE)
